import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 20.0                 # outer radius of the sleeve
L = 44.5                 # overall length (axis along Y)
T_PLATE = 1.6            # thickness of the front end plate
R_BORE = 18.5            # main bore radius
R_BACK = 17.85           # inner radius of the short section at the open (back) end
D_BACK = 2.9             # depth of that section
KEY_W = 1.6              # width of the two keys at the open end (+X / -X)
KEY_PROTRUDE = 0.3       # how far the keys stand proud of the smaller radius

# front-plate latch pattern (in the XZ plane, front view)
R_SLOT_IN = 0.525 * R    # inner radius of the C-slot
R_SLOT_OUT = 0.70 * R    # outer radius of the C-slot
GAP_HALF = 0.186 * R     # half width of the top bridge between slot ends
BLOB_CX = -0.464 * R     # lobe centre (X)
BLOB_CZ = -0.385 * R     # lobe centre (Z)
BLOB_R = 0.276 * R       # lobe radius
FILLET_IN = 3.0          # fillet where lobe meets the inner slot edge
FILLET_OUT = 2.0         # fillet where lobe meets the outer slot edge
HOLE_R = 0.151 * R       # central hole radius

# long side slot (on -X side)
SIDE_SLOT_W = 2.2
SIDE_SLOT_Z = 0.1
SIDE_SLOT_HALF_LEN = 18.0
# two shallow guide grooves on the inside of the -X wall, flanking the slot
GROOVES = ((1.9, 3.0), (-5.4, -3.4))   # (z_low, z_high) of each groove
GROOVE_DEPTH = 0.5

# vent slits (on +X lower side): three obround cuts normal to the surface
SLIT_ANGLES = (-38.8, -45.3, -51.8)
SLIT_W = 1.0
SLIT_LEN = 7.0
SLIT_Y = -0.8

Y0 = -L / 2.0            # front face
Y1 = L / 2.0             # open back end


def xz_wp(y, seam_deg=0.0):
    """Workplane parallel to XZ at height y; extrusions go toward -Y.
    seam_deg sets where full circles drawn on it start (their seam line)."""
    a = math.radians(seam_deg)
    pl = cq.Plane(origin=(0, y, 0), xDir=(math.cos(a), 0, math.sin(a)), normal=(0, -1, 0))
    return cq.Workplane(pl)


# ---------------- main body ----------------
body = xz_wp(Y1, 230.0).circle(R).extrude(L)
bore = xz_wp(Y1 - D_BACK, 90.0).circle(R_BORE).extrude(L - T_PLATE - D_BACK)
back = xz_wp(Y1 + 0.5, 90.0).circle(R_BACK).extrude(D_BACK + 0.5)
body = body.cut(bore).cut(back)

# two small keys at the open end (+X and -X)
r_small = min(R_BORE, R_BACK) - KEY_PROTRUDE
key_len = R - 0.5 - r_small
for sgn in (1.0, -1.0):
    key = (cq.Workplane("XY")
           .box(key_len, D_BACK, KEY_W)
           .translate((sgn * (r_small + key_len / 2.0), Y1 - D_BACK / 2.0, 0)))
    body = body.union(key)

# ---------------- front plate pattern ----------------
ext = T_PLATE + 2.0
ring = xz_wp(Y0 + T_PLATE + 1.0).circle(R_SLOT_OUT).circle(R_SLOT_IN).extrude(ext)
gap = (cq.Workplane("XY")
       .box(2 * GAP_HALF, ext + 2, R)
       .translate((0, Y0 + T_PLATE / 2.0, R / 2.0)))
ring = ring.cut(gap)
blob = xz_wp(Y0 + T_PLATE + 1.0).center(BLOB_CX, BLOB_CZ).circle(BLOB_R).extrude(ext)
void = ring.union(blob)
body = body.cut(void)


def circle_hits(r1, cx, cz, r2):
    d = math.hypot(cx, cz)
    a = (r1 * r1 - r2 * r2 + d * d) / (2 * d)
    h = math.sqrt(max(r1 * r1 - a * a, 0.0))
    ux, uz = cx / d, cz / d
    px, pz = a * ux, a * uz
    return [(px - h * uz, pz + h * ux), (px + h * uz, pz - h * ux)]


class NearPts(cq.Selector):
    """Edges whose centre lies near one of the given (x, z) points, inside the front plate."""

    def __init__(self, pts, tol=0.3):
        self.pts = pts
        self.tol = tol

    def filter(self, objs):
        out = []
        for o in objs:
            c = o.Center()
            for (x, z) in self.pts:
                if abs(c.x - x) < self.tol and abs(c.z - z) < self.tol and c.y < Y0 + T_PLATE + 0.01:
                    out.append(o)
                    break
        return out


# round the corners where the lobe meets the C-slot
body = body.edges("|Y").edges(NearPts(circle_hits(R_SLOT_IN, BLOB_CX, BLOB_CZ, BLOB_R))).fillet(FILLET_IN)
body = body.edges("|Y").edges(NearPts(circle_hits(R_SLOT_OUT, BLOB_CX, BLOB_CZ, BLOB_R))).fillet(FILLET_OUT)

# central hole in the latch tongue
hole = xz_wp(Y0 + T_PLATE + 1.0).circle(HOLE_R).extrude(ext)
body = body.cut(hole)

# ---------------- long side slot on -X ----------------
side_slot = (cq.Workplane("XY")
             .box(R - min(R_BORE, R_BACK) + 2.0, 2 * SIDE_SLOT_HALF_LEN, SIDE_SLOT_W)
             .translate((-(min(R_BORE, R_BACK) + R) / 2.0, 0, SIDE_SLOT_Z)))
body = body.cut(side_slot)

# guide grooves along the inside of the -X wall (from the end plate to the lip)
g_len = (Y1 - D_BACK) - (Y0 + T_PLATE)
for (z_lo, z_hi) in GROOVES:
    zc = 0.5 * (z_lo + z_hi)
    x_in = math.sqrt(R_BORE ** 2 - max(abs(z_lo), abs(z_hi)) ** 2)
    groove = (cq.Workplane("XY")
              .box(R_BORE + GROOVE_DEPTH - x_in + 1.0, g_len, z_hi - z_lo)
              .translate((-(x_in - 1.0 + R_BORE + GROOVE_DEPTH) / 2.0,
                          (Y0 + T_PLATE + Y1 - D_BACK) / 2.0, zc)))
    ring_keep = xz_wp(Y1, 90.0).circle(R + 1.0).circle(R_BORE + GROOVE_DEPTH).extrude(L)
    body = body.cut(groove.cut(ring_keep))

# ---------------- vent slits on +X lower side ----------------
for a in SLIT_ANGLES:
    slit = (cq.Workplane("YZ", origin=(R - 4.0, 0, 0))
            .center(SLIT_Y, 0)
            .slot2D(SLIT_LEN, SLIT_W, 0)
            .extrude(8.0)                                   # radial along +X
            .rotate((0, 0, 0), (0, 1, 0), -a))              # turn to angle a in XZ
    body = body.cut(slit)

result = body
